import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 260.0          # outer length (X)
W = 160.6          # outer width (Y)
H = 34.0           # overall height (Z)
R_V = 3.5          # outer vertical corner radius
R_TOP = 3.0        # outer top edge fillet
R_BOT = 3.0        # outer bottom edge fillet
T_WALL_X = 6.9     # end wall thickness (+/-X walls)
T_WALL_Y = 6.3     # side wall thickness (+/-Y walls)
R_IN = 1.0         # inner vertical corner radius of the cavity

LEDGE_H = 12.2     # top face of the bottom ledge (bezel)
R_OPEN = 1.3       # round on the opening's top edge
OPEN_X = 17.2      # window inset from the outer faces at +/-X
OPEN_YF = 12.9     # window inset at -Y (front)
OPEN_YB = 11.3     # window inset at +Y (back)
REB_W = 2.9        # rebate around the window on the underside
REB_H = 1.5

HOLE_D = 5.3       # blind screw holes in the ledge corners
HOLE_DEPTH = 6.0
HOLE_IN_X = 11.7   # hole centre inset from the outer faces
HOLE_IN_Y = 11.0

SLOT_W = 27.3      # rectangular slots through the walls
SLOT_H = 14.0      # slot floor is flush with the ledge top
SLOT_R = 2.0
SLOT_FRONT_X = 85.0   # slot in the -Y wall
SLOT_LEFT_Y = 0.5     # slot in the -X wall
SLOT_EDGE_R = 1.0     # round on the slots' outer edges

REC_X0 = -38.0     # flex-cable recess along the +Y ledge
REC_END = 1.5      # recess stops this far short of the window's +X end
REC_Z = 6.2        # floor of the recess
REC_INTO_WALL = 0.4
REC_TOP = 0.3      # recess reaches this far above the ledge top

TEXT = "TJC1060X570-011GS-1"
TEXT_CAP = 13.2    # cap height of the raised part number
TEXT_LEN = 191.0   # overall length of the part number
TEXT_H = 0.6       # emboss height
TEXT_Z0 = 9.6      # z of the cap tops (text reads with the part turned over)

# ---------------- body ----------------
body = (
    cq.Workplane("XY")
    .box(L, W, H, centered=(True, True, False))
    .edges("|Z").fillet(R_V)
    .faces(">Z").edges().fillet(R_TOP)
    .faces("<Z").edges().fillet(R_BOT)
)

# cavity above the ledge
cavity = (
    cq.Workplane("XY", origin=(0, 0, LEDGE_H))
    .rect(L - 2 * T_WALL_X, W - 2 * T_WALL_Y)
    .extrude(H)
    .edges("|Z").fillet(R_IN)
)
body = body.cut(cavity)

# display window through the ledge
ox0, ox1 = -L / 2 + OPEN_X, L / 2 - OPEN_X
oy0, oy1 = -W / 2 + OPEN_YF, W / 2 - OPEN_YB
ocx, ocy = (ox0 + ox1) / 2, (oy0 + oy1) / 2
opening = (
    cq.Workplane("XY", origin=(ocx, ocy, -1))
    .rect(ox1 - ox0, oy1 - oy0)
    .extrude(LEDGE_H + 2)
)
body = body.cut(opening)

# recess in the +Y ledge (flex cable clearance), cut slightly into the wall
rx0, rx1 = REC_X0, ox1 - REC_END
ry0, ry1 = oy1 - 1.0, W / 2 - T_WALL_Y + REC_INTO_WALL
recess = (
    cq.Workplane("XY", origin=((rx0 + rx1) / 2, (ry0 + ry1) / 2, REC_Z))
    .rect(rx1 - rx0, ry1 - ry0)
    .extrude(LEDGE_H + REC_TOP - REC_Z)
)
body = body.cut(recess)


# round the top edges of the window (incl. the recess step)
def _window_top_edge(e):
    bb = e.BoundingBox()
    inside = (ox0 - 0.1 <= bb.xmin and bb.xmax <= ox1 + 0.1
              and oy0 - 0.1 <= bb.ymin and bb.ymax <= oy1 + 0.1)
    return inside and bb.zmin > REC_Z - 0.1 and bb.zmax < LEDGE_H + 0.1


body = body.newObject([e for e in body.edges().vals() if _window_top_edge(e)]).fillet(R_OPEN)

# rebate around the window on the underside (for a cover glass)
rebate = (
    cq.Workplane("XY", origin=(ocx, ocy, -1))
    .rect(ox1 - ox0 + 2 * REB_W, oy1 - oy0 + 2 * REB_W)
    .extrude(REB_H + 1)
)
body = body.cut(rebate)

# blind screw holes in the ledge corners
hx, hy = L / 2 - HOLE_IN_X, W / 2 - HOLE_IN_Y
holes = (
    cq.Workplane("XY", origin=(0, 0, LEDGE_H - HOLE_DEPTH))
    .pushPoints([(hx, hy), (-hx, hy), (hx, -hy), (-hx, -hy)])
    .circle(HOLE_D / 2)
    .extrude(HOLE_DEPTH + 1)
)
body = body.cut(holes)

# slots through the walls, floor flush with the ledge top, outer edge rounded
slot_zc = LEDGE_H + SLOT_H / 2
slot_f = (
    cq.Workplane("XZ", origin=(SLOT_FRONT_X, -W / 2 + T_WALL_Y + 1, slot_zc))
    .rect(SLOT_W, SLOT_H)
    .extrude(T_WALL_Y + 3)
    .edges("|Y").fillet(SLOT_R)
)
slot_l = (
    cq.Workplane("YZ", origin=(-L / 2 - 1, SLOT_LEFT_Y, slot_zc))
    .rect(SLOT_W, SLOT_H)
    .extrude(T_WALL_X + 3)
    .edges("|X").fillet(SLOT_R)
)
body = body.cut(slot_f).cut(slot_l)


def _slot_outer_edge(e):
    bb = e.BoundingBox()
    in_z = bb.zmin > LEDGE_H - 0.5 and bb.zmax < LEDGE_H + SLOT_H + 0.5
    front = (bb.ymax < -W / 2 + 0.01 and bb.xmin > SLOT_FRONT_X - SLOT_W / 2 - 0.5
             and bb.xmax < SLOT_FRONT_X + SLOT_W / 2 + 0.5)
    left = (bb.xmax < -L / 2 + 0.01 and bb.ymin > SLOT_LEFT_Y - SLOT_W / 2 - 0.5
            and bb.ymax < SLOT_LEFT_Y + SLOT_W / 2 + 0.5)
    return in_z and (front or left)


body = body.newObject([e for e in body.edges().vals() if _slot_outer_edge(e)]).fillet(SLOT_EDGE_R)

# raised part number on the +Y face; it reads upright with the part turned over
def _part_number():
    size = TEXT_CAP / 0.729                   # cap height of the default sans font
    raw = cq.Workplane("XY").text(TEXT, size, TEXT_H, halign="center", valign="bottom").val()
    sx = TEXT_LEN / raw.BoundingBox().xlen    # condense to the marked length
    raw = raw.transformGeometry(cq.Matrix([[sx, 0, 0, 0], [0, 1, 0, 0], [0, 0, 1, 0]]))
    # local text frame: x -> +X, text up (+y) -> -Z, extrusion (+z) -> +Y (outwards)
    plane = cq.Plane(origin=(0, W / 2 - 0.05, TEXT_Z0 + TEXT_CAP), xDir=(1, 0, 0), normal=(0, 1, 0))
    return raw.moved(cq.Location(plane))


try:
    body = body.union(_part_number())
except Exception:   # no usable font: keep the plain frame
    pass

result = body
